import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Hinged instrument box: base with a moulded instrument tray (left, -Y side)
# and the open lid lying flat behind it (+Y side), joined by two 3-knuckle
# hinges along X.
# ---------------------------------------------------------------------------

# overall box (base and lid share the same footprint)
L = 160.0          # length along X
W = 101.0          # depth along Y
H = 33.0           # height of base body / lid
C = 5.0            # chamfer of vertical and bottom edges
GAP = 13.5         # hinge gap between base back face and lid front face

# tray on top of the base
TRAY_H = 13.5      # tray height above base top
TRAY_IN_B = 5.0    # inset of tray foot from base outline
TRAY_IN_T = 6.0    # inset of tray top from base outline (draft)
TRAY_CH_B = 4.5    # corner chamfer of tray foot
TRAY_CH_T = 2.0    # corner chamfer of tray top
TRAY_FIL = 2.0     # fillet on tray top outer edge

# big trough (axis along X) over the compartment and the long slots
SCOOP_HALF = 31.0          # half width where the trough leaves the top
SCOOP_DEPTH = 7.0
SCOOP_RB = 5.0             # convex blend radius at the rims

# left compartment
COMP_X0, COMP_X1 = 9.5, 36.3   # from the -X end
COMP_LEN_Y = 82.0
COMP_FLOOR = 4.0

# long slots
LS_N = 6
LS_X0 = 42.6                   # first slot centre from -X end
LS_PITCH = 13.4
LS_W = 5.8
LS_LEN = 76.0
LS_FLOOR = 8.0

# small trough (axis along Y) with the small instrument grooves
SS_CX = 134.7                  # centre from -X end
SS_HALF = 12.5
SS_DEPTH = 2.2
SS_RB = 4.0
SS_N = 8
SS_PITCH = 10.43
SS_X0, SS_X1 = 119.8, 148.3    # slot extent from -X end
SS_W = 3.2
SS_GROOVE = 1.2                # groove depth below the trough surface
SS_RUNOUT = 0.3                # groove floor meets the top this far from its -X end
SS_RAMP = 0.45                 # slope of the run-out ramp at the -X end

# shallow recess in the underside of the base near the front edge
REC_W, REC_D = 24.0, 5.0

# latch on the tray front
LATCH_W = 22.0     # outer width of the latch (tongue + side slits)
TONGUE_T = 2.5     # tongue thickness
TONGUE_Y = 4.2     # tongue face distance from the base front face
SLIT_W = 1.3       # width of the U-slit around the tongue
CATCH_H = 4.2      # height of the catch ridge
CATCH_Y = 2.6      # catch apex distance from the base front face

# lid
WALL = 4.0         # lid side wall thickness
FLOOR_T = 3.0      # lid floor thickness
IN_CH = 2.1        # inner vertical corner chamfer
FLOOR_CH = 3.0     # inner floor chamfer
RIM_CH = 0.8       # chamfer on the inner rim edge
RAMP_D, RAMP_H = 1.3, 7.0      # lead-in ramp above the latch pocket
WIN_W = 21.0
WIN_Z0, WIN_Z1 = 18.3, 22.5    # latch window in lid +Y wall
BOSS_W, BOSS_H, BOSS_P = 25.0, 5.6, 1.75
WIN_SKIN = 0.8                 # material left at the bottom of the latch pocket

# hinge
HX_R = 5.5                     # knuckle radius
HX_Z = H - 0.3                 # hinge axis height
LEAF_Z = 18.4                  # lowest point of leaf on box face
HINGE_SPANS = [(12.0, 43.0), (117.0, 148.0)]  # from -X end
KN_GAP = 0.5

# derived
YB0, YB1 = -GAP / 2 - W, -GAP / 2      # base Y range
YL0, YL1 = GAP / 2, GAP / 2 + W        # lid Y range
YBC = (YB0 + YB1) / 2
YLC = (YL0 + YL1) / 2
HT = H + TRAY_H
X0 = -L / 2


def chamfered_box(lx, ly, lz, cx, cy, z0, c):
    b = cq.Workplane("XY").box(lx, ly, lz, centered=(True, True, False))
    b = b.translate((cx, cy, z0))
    b = b.edges("|Z").chamfer(c)
    b = b.faces("<Z").edges().chamfer(c)
    return b


def chamf_rect_pts(lx, ly, c):
    a, b = lx / 2, ly / 2
    return [(-a + c, -b), (a - c, -b), (a, -b + c), (a, b - c),
            (a - c, b), (-a + c, b), (-a, b - c), (-a, -b + c)]


def dip_profile_z(u, top, depth, half, rb):
    """Trough profile: concave arc blended tangentially into the flat top
    with convex arcs of radius rb (|u| <= half)."""
    S = (half ** 2 + depth ** 2) / (2.0 * depth)      # rb + rc
    rc = S - rb
    ut = half - rb * half / S
    u = abs(u)
    if u >= half:
        return top
    if u <= ut:
        return top - depth + rc - math.sqrt(rc ** 2 - u ** 2)
    return top - rb + math.sqrt(rb ** 2 - (half - u) ** 2)


def dip_cutter(plane, uc, top, depth, half, rb, x0, length):
    """Cutter for a smooth trough, drawn in `plane` (local u = across the
    trough, v = up) as one spline with horizontal end tangents, extruded
    `length` from workplane offset x0."""
    us = [-0.78, -0.5, -0.25, 0.0, 0.25, 0.5, 0.78]
    pts = [(k * half, dip_profile_z(k * half, top, depth, half, rb)) for k in us]
    pts.append((half, top))
    ext = 4.0
    wp = (cq.Workplane(plane).workplane(offset=x0).center(uc, 0)
          .moveTo(-half - ext, top + ext).lineTo(-half - ext, top)
          .lineTo(-half, top)
          .spline(pts, tangents=[(1, 0), (1, 0)], includeCurrent=True)
          .lineTo(half + ext, top).lineTo(half + ext, top + ext).close())
    return wp.extrude(length)


# ---------------------------------------------------------------- base body
base = chamfered_box(L, W, H, 0, YBC, 0, C)

# tray: ruled loft between chamfered rectangles (drafted walls)
pb = chamf_rect_pts(L - 2 * TRAY_IN_B, W - 2 * TRAY_IN_B, TRAY_CH_B)
pt = chamf_rect_pts(L - 2 * TRAY_IN_T, W - 2 * TRAY_IN_T, TRAY_CH_T)
tray = (cq.Workplane("XY").workplane(offset=H).center(0, YBC)
        .polyline(pb).close()
        .workplane(offset=TRAY_H).polyline(pt).close()
        .loft(ruled=True))
for _r in (TRAY_FIL, TRAY_FIL * 0.75, TRAY_FIL * 0.5):
    try:
        tray = tray.faces(">Z").edges().fillet(_r)
        break
    except Exception:
        pass
base = base.union(tray)

# big trough (axis X), ends at the +X wall of the last long slot
scoop_x1 = X0 + LS_X0 + (LS_N - 1) * LS_PITCH + LS_W / 2
scoop = dip_cutter("YZ", YBC, HT, SCOOP_DEPTH, SCOOP_HALF, SCOOP_RB,
                   X0 - 2, scoop_x1 - (X0 - 2))
base = base.cut(scoop)

# compartment
comp = (cq.Workplane("XY").box(COMP_X1 - COMP_X0, COMP_LEN_Y, HT,
                               centered=(True, True, False))
        .translate((X0 + (COMP_X0 + COMP_X1) / 2, YBC, COMP_FLOOR)))
base = base.cut(comp)

# long slots
for i in range(LS_N):
    cx = X0 + LS_X0 + i * LS_PITCH
    s = (cq.Workplane("XY").box(LS_W, LS_LEN, HT, centered=(True, True, False))
         .translate((cx, YBC, LS_FLOOR)))
    base = base.cut(s)

# small trough (axis Y) through the whole tray depth
scoop2 = dip_cutter("XZ", X0 + SS_CX, HT, SS_DEPTH, SS_HALF, SS_RB,
                    -(YB0 - 2), -(W + 4))
base = base.cut(scoop2)

# small slots: shallow grooves of constant depth under the small trough;
# at their -X end the floor ramps up and runs out on the top face
groove_zone = dip_cutter("XZ", X0 + SS_CX, HT - SS_GROOVE, SS_DEPTH, SS_HALF,
                         SS_RB, -(YB0 - 2), -(W + 4))
gx0 = X0 + SS_X0 + SS_RUNOUT
gx1 = X0 + SS_X1
ss_y0 = YBC - (SS_N - 1) / 2 * SS_PITCH
ramp_in = (cq.Workplane("XZ").workplane(offset=-(YB0 - 2))
           .polyline([(gx0 - 3.0, HT + 3.0),
                      (gx0 - 3.0, HT + 3.0 * SS_RAMP),
                      (gx1 + 1.0, HT - SS_RAMP * (gx1 + 1.0 - gx0)),
                      (gx1 + 1.0, HT + 3.0)])
           .close().extrude(-(W + 4)))
gz = groove_zone.intersect(ramp_in)
for i in range(SS_N):
    cy = ss_y0 + i * SS_PITCH
    ln = SS_X1 - SS_X0
    s = (cq.Workplane("XY").workplane(offset=HT - SS_DEPTH - SS_GROOVE - 1.0)
         .center(X0 + (SS_X0 + SS_X1) / 2, cy)
         .slot2D(ln, SS_W).extrude(SS_DEPTH + SS_GROOVE + 3.0))
    base = base.cut(s.intersect(gz))

# latch: a flexible tongue in the tray front, freed by a U-shaped slit,
# with a ridge-shaped catch on its top protruding beyond the tray face
y_tf = YB0 + TONGUE_Y                     # tongue face (vertical)
y_tb = y_tf + TONGUE_T                    # tongue back
cw = LATCH_W - 2 * SLIT_W                 # tongue width
uslot = (cq.Workplane("XY").box(LATCH_W, y_tb + SLIT_W - (YB0 - 1), TRAY_H + 2,
                                centered=(True, False, False))
         .translate((0, YB0 - 1, H)))
base = base.cut(uslot)
tongue = (cq.Workplane("XY").box(cw, TONGUE_T, TRAY_H + 0.5,
                                 centered=(True, False, False))
          .translate((0, y_tf, H - 0.5)))
base = base.union(tongue)
y_apex = YB0 + CATCH_Y
catch = (cq.Workplane("YZ").workplane(offset=-cw / 2)
         .polyline([(y_tf + 0.5, HT), (y_apex, HT - CATCH_H / 2),
                    (y_tf + 0.5, HT - CATCH_H)]).close().extrude(cw))
trap = (cq.Workplane("XY").workplane(offset=HT - CATCH_H - 1)
        .polyline([(-cw / 2, y_tf + 0.5), (cw / 2, y_tf + 0.5),
                   (cw / 2 - 2.2, y_apex), (-cw / 2 + 2.2, y_apex)])
        .close().extrude(CATCH_H + 2))
catch = catch.intersect(trap)
base = base.union(catch)

# shallow recess on the underside near the front edge
rec = (cq.Workplane("XY").box(REC_W, REC_D, 2.0, centered=(True, False, True))
       .translate((0, YB0 + C + 0.5, 0)))
base = base.cut(rec)

# ---------------------------------------------------------------- lid
lid = chamfered_box(L, W, H, 0, YLC, 0, C)
cav = (cq.Workplane("XY").box(L - 2 * WALL, W - 2 * WALL, H,
                              centered=(True, True, False))
       .translate((0, YLC, FLOOR_T)))
cav = cav.edges("|Z").chamfer(IN_CH)
cav = cav.faces("<Z").edges().chamfer(FLOOR_CH)
lid = lid.cut(cav)

# small 45 deg chamfer on the inner rim edge (flared ruled loft cutter)
pin = chamf_rect_pts(L - 2 * WALL, W - 2 * WALL, IN_CH)
pout = chamf_rect_pts(L - 2 * WALL + 2 * (RIM_CH + 1), W - 2 * WALL + 2 * (RIM_CH + 1),
                      IN_CH + (2 - math.sqrt(2)) * (RIM_CH + 1))
flare = (cq.Workplane("XY").workplane(offset=H - RIM_CH).center(0, YLC)
         .polyline(pin).close()
         .workplane(offset=RIM_CH + 1).polyline(pout).close()
         .loft(ruled=True))
lid = lid.cut(flare)

# lead-in ramp on the inside of the +Y wall above the latch pocket
ramp = (cq.Workplane("YZ").workplane(offset=-WIN_W / 2)
        .polyline([(YL1 - WALL - 0.5, H + 0.5), (YL1 - WALL + RAMP_D, H + 0.5),
                   (YL1 - WALL + RAMP_D, H), (YL1 - WALL, H - RAMP_H),
                   (YL1 - WALL - 0.5, H - RAMP_H)])
        .close().extrude(WIN_W))
lid = lid.cut(ramp)

# latch boss on the outside of the lid +Y wall, latch pocket behind it
boss = (cq.Workplane("XZ").workplane(offset=-YL1)
        .center(0, (WIN_Z0 + WIN_Z1) / 2)
        .slot2D(BOSS_W, BOSS_H).extrude(-BOSS_P))
try:
    boss = boss.faces(">Y").edges().fillet(BOSS_P * 0.95)
except Exception:
    pass
lid = lid.union(boss)
win_depth = WALL + BOSS_P - WIN_SKIN        # blind pocket from the inside
win = (cq.Workplane("XY").box(WIN_W, win_depth + 1.0, WIN_Z1 - WIN_Z0,
                              centered=(True, False, False))
       .translate((0, YL1 - WALL - 1.0, WIN_Z0)))
lid = lid.cut(win)

# ---------------------------------------------------------------- hinges
def make_knuckle(side, x0, x1):
    """Hinge knuckle: barrel of radius HX_R on the hinge axis plus a leaf
    joining it to the box face.  side = -1 -> base, +1 -> lid."""
    yf = side * GAP / 2
    # lower tangent from the leaf root (on the box face) to the barrel
    py, pz = yf, LEAF_Z
    dx, dz = -py, HX_Z - pz
    d = math.hypot(dx, dz)
    a = math.atan2(dz, dx)
    b = math.asin(HX_R / d)
    ang = a - b if side < 0 else a + b
    tl = d * math.cos(b)
    ty, tz = py + tl * math.cos(ang), pz + tl * math.sin(ang)
    # barrel meets the box-top level on the face side
    uy = side * math.sqrt(HX_R ** 2 - (H - HX_Z) ** 2)
    wp = (cq.Workplane("YZ").workplane(offset=x0)
          .moveTo(py, pz).lineTo(ty, tz)
          .threePointArc((0, HX_Z + HX_R), (uy, H))
          .lineTo(yf, H).close())
    return wp.extrude(x1 - x0)


hinges = None
for (s0, s1) in HINGE_SPANS:
    seg = (s1 - s0) / 3.0
    for k in range(3):
        side = -1 if k == 1 else 1     # outer knuckles: lid, middle: base
        xa = X0 + s0 + k * seg + (KN_GAP / 2 if k > 0 else 0)
        xb = X0 + s0 + (k + 1) * seg - (KN_GAP / 2 if k < 2 else 0)
        kn = make_knuckle(side, xa, xb)
        hinges = kn if hinges is None else hinges.union(kn)

result = base.union(lid).union(hinges)

VIEW = {"azimuth": 45, "elevation": 26}
